import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
LEN_X = 100.0        # overall width  (X)
LEN_Y = 176.0        # overall length (Y)
HEIGHT = 32.0        # overall height (Z)
WALL = 3.0           # side wall thickness (all four walls)
FLOOR = 6.0          # top of the floor ledge above the base
LEDGE = 7.6          # ledge width between inner wall face and floor pocket
POCKET_DEPTH = 3.1   # depth of the recessed floor pocket below the ledge
NOTCH_R = 6.0        # concave (inverted) corner radius of the floor pocket
HOLE_W = 18.0        # rectangular window in the +X wall, length along Y
HOLE_H = 12.0        # window height (Z)
HOLE_Y = 0.0         # window centre along Y
HOLE_Z = 16.0        # window centre height above the base

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived sizes ----------------
IN_X = LEN_X - 2 * WALL          # cavity size
IN_Y = LEN_Y - 2 * WALL
PK_X = IN_X - 2 * LEDGE          # floor pocket size (before corner notches)
PK_Y = IN_Y - 2 * LEDGE

# ---------------- outer block ----------------
body = cq.Workplane("XY").box(LEN_X, LEN_Y, HEIGHT, centered=(True, True, False))

# ---------------- open-top cavity down to the floor ledge ----------------
cavity = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR)
    .rect(IN_X, IN_Y)
    .extrude(HEIGHT - FLOOR + 1.0)
)
body = body.cut(cavity)

# ---------------- recessed floor pocket with concave corner notches ----------------
# rectangle minus a quarter-circle at every corner -> "ticket" shaped pocket
pocket = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR - POCKET_DEPTH)
    .rect(PK_X, PK_Y)
    .extrude(POCKET_DEPTH + 1.0)
)
corner_pts = [(sx * PK_X / 2, sy * PK_Y / 2) for sx in (-1, 1) for sy in (-1, 1)]
notches = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR - POCKET_DEPTH - 1.0)
    .pushPoints(corner_pts)
    .circle(NOTCH_R)
    .extrude(POCKET_DEPTH + 3.0)
)
pocket = pocket.cut(notches)
body = body.cut(pocket)

# ---------------- rectangular window through the +X wall ----------------
window = (
    cq.Workplane("YZ")
    .workplane(offset=LEN_X / 2 - WALL - 1.0)
    .center(HOLE_Y, HOLE_Z)
    .rect(HOLE_W, HOLE_H)
    .extrude(WALL + 2.0)
)
body = body.cut(window)

result = body
